import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Small revolver, lying flat: side profile in the XY plane (+X = muzzle,
# +Y = top of the gun), thickness along Z.  Layout is sketched in "px"
# units of a side-profile drawing and scaled by S to millimetres.
# ---------------------------------------------------------------------------
S = 0.7                      # mm per drawing unit
U0, V0 = 144.6, 350.0        # drawing point that maps to the origin (cylinder centre)

# driving dimensions (drawing units)
FRAME_T2 = 8.5               # half thickness of the frame plate
GRIP_T2 = 16.9               # half thickness of grip (frame + panels)
PANEL_FILLET = 2.7           # rounding of the grip panel faces
CYL_R = 22.8                 # cylinder radius
CYL_U0, CYL_U1 = 121.5, 167.7
CYL_AXIS_V = 350.0
N_CHAMBERS = 8
CYL_FRONT_CH, CYL_REAR_CH = 2.0, 1.2
FLUTE_W = 6.0               # flute width
FLUTE_DEPTH = 2.4
FLUTE_U0 = 133.0
BARREL_AP = 9.4              # barrel apothem (octagonal barrel)
BARREL_AXIS_V = 331.9
BARREL_U0, BARREL_U1 = 168.0, 248.5
BORE_R = 6.6
SHROUD_R = 11.2
ROD_R = 5.2
ROD_U0, ROD_U1 = 184.4, 218.5
WIN_U0, WIN_U1, WIN_V0, WIN_V1 = 111.1, 168.5, 323.5, 374.6
SCREW_R, CSK_R, CSK_DEPTH = 2.0, 7.4, 4.0    # grip screw hole / countersink radius


def P(u, v):
    return ((u - U0) * S, (V0 - v) * S)


def X(u):
    return (u - U0) * S


def Yv(v):
    return (V0 - v) * S


def L(d):
    return d * S


def profile(segments):
    """segments: list of ('l', [(u,v),...]) or ('s', [(u,v),...]) drawing a closed wire"""
    first = segments[0][1][0]
    wp = cq.Workplane("XY").moveTo(*P(*first))
    started = False
    for kind, pts in segments:
        pp = [P(*p) for p in pts]
        if not started:
            pp = pp[1:]
            started = True
        if kind == "l":
            for p in pp:
                wp = wp.lineTo(*p)
        else:
            wp = wp.spline(pp, includeCurrent=True)
    return wp.close()


# ---------------------------------------------------------------- frame plate
frame_segments = [
    ("l", [(17.5, 466.8)]),
    ("s", [(13.2, 465.3), (11.7, 460.5), (14.7, 444.0), (21.2, 422.7), (28.6, 406.3), (37.6, 390.0), (46.5, 376.0), (55.5, 365.0)]),
    ("s", [(66.9, 360.3), (77.7, 355.6), (86.4, 347.5), (93.2, 339.4), (96.6, 331.5), (98.0, 323.3)]),
    ("l", [(98.0, 312.3), (128.5, 312.3), (128.5, 316.2), (174.6, 316.2), (174.6, 320.8),
           (184.4, 320.8), (184.4, 357.0), (181.5, 361.0), (181.5, 386.0), (173.8, 389.0),
           (169.5, 391.0), (169.5, 402.0), (111.3, 402.0), (109.8, 398.0), (106.9, 393.5), (100.6, 389.4), (97.7, 390.6), (98.5, 394.6)]),
    ("s", [(96.4, 396.5), (88.3, 399.8), (81.7, 406.3), (76.8, 414.5), (74.4, 422.7), (72.7, 439.0),
           (76.0, 455.4), (77.3, 461.0), (76.2, 465.3), (72.0, 466.8)]),
]
frame = profile(frame_segments).extrude(L(FRAME_T2), both=True)

# cylinder window
win = (cq.Workplane("XY")
       .center(X((WIN_U0 + WIN_U1) / 2), Yv((WIN_V0 + WIN_V1) / 2))
       .rect(L(WIN_U1 - WIN_U0), L(WIN_V1 - WIN_V0))
       .extrude(L(30), both=True))
frame = frame.cut(win)

# trigger guard: rounded loop, slightly ridged outer face, stepped opening with a thin web
TG_OUT_U0, TG_OUT_U1, TG_OUT_V1, TG_OUT_R = 111.5, 169.5, 432.0, 16.0
TG_U0, TG_U1, TG_V0, TG_V1, TG_R = 115.3, 165.8, 393.2, 427.8, 11.5
TG_TAPER_OUT = 5.0           # deg, draft of the outer face from the mid-plane ridge
TG_LEDGE = 1.6               # width of the web ledge inside the loop
TG_WEB_T2 = 1.2              # half thickness of the web


def rrect_sketch(u0, u1, v0, v1, r, z=0.0):
    w, h = L(u1 - u0), L(v1 - v0)
    return (cq.Workplane("XY", origin=(0, 0, z))
            .center(X((u0 + u1) / 2), Yv((v0 + v1) / 2))
            .sketch().rect(w, h).vertices().fillet(L(r)).finalize())


guard = None
for sgn in (1, -1):
    g = (rrect_sketch(TG_OUT_U0, TG_OUT_U1, 382.0, TG_OUT_V1, TG_OUT_R)
         .extrude(sgn * L(FRAME_T2), taper=TG_TAPER_OUT))
    guard = g if guard is None else guard.union(g)
frame = frame.union(guard)
frame = frame.cut(rrect_sketch(TG_U0, TG_U1, TG_V0, TG_V1, TG_R, -L(15)).extrude(L(30)))
for sgn in (1, -1):
    o1 = (rrect_sketch(TG_U0 - TG_LEDGE, TG_U1 + TG_LEDGE, TG_V0 - TG_LEDGE, TG_V1 + TG_LEDGE,
                       TG_R + TG_LEDGE, sgn * L(TG_WEB_T2))
          .extrude(sgn * L(12)))
    frame = frame.cut(o1)

# sloped ramp on the frame between the cylinder window and the trigger guard
RAMP_Z_LOW = 2.5                 # height of the ramp at the guard opening edge
ramp_pts = [(WIN_U0, WIN_V1), (WIN_U1, WIN_V1), (TG_U1, TG_V0), (149.0, TG_V0)]
ramp_prism = (cq.Workplane("XY", origin=(0, 0, -L(1)))
              .polyline([P(*p) for p in ramp_pts]).close().extrude(L(20)))
pa = cq.Vector(X(WIN_U0), Yv(WIN_V1), L(FRAME_T2))
pc = cq.Vector(X(WIN_U0), Yv(TG_V0), L(RAMP_Z_LOW))
nrm = cq.Vector(1, 0, 0).cross(pc - pa).normalized()
if nrm.z < 0:
    nrm = nrm * -1
half = (cq.Workplane(cq.Plane(origin=pa, xDir=cq.Vector(1, 0, 0), normal=nrm))
        .rect(L(400), L(400)).extrude(L(60)))
frame = frame.cut(ramp_prism.intersect(half))

# ------------------------------------------------------------ grip panels
panel_segments = [
    ("l", [(19.0, 465.3)]),
    ("s", [(14.8, 463.8), (13.2, 459.0), (16.2, 444.0), (22.6, 423.0), (30.0, 406.6), (39.0, 390.6), (47.6, 377.0), (56.0, 366.6)]),
    ("s", [(67.0, 366.8), (79.0, 372.6), (86.0, 376.8), (92.0, 381.2), (96.4, 386.4), (97.9, 390.4)]),
    ("l", [(97.3, 393.6)]),
    ("s", [(95.2, 395.2), (87.8, 398.4), (80.6, 405.4), (75.4, 414.3), (73.0, 422.7), (71.3, 439.0),
           (74.5, 455.4), (75.7, 460.0), (74.6, 463.8), (70.5, 465.3)]),
]
grip = profile(panel_segments).extrude(L(GRIP_T2), both=True)
grip = grip.faces(">Z or <Z").edges().fillet(L(PANEL_FILLET))

# countersunk screws on the upper panel only
for (u, v) in [(55.6, 412.0), (41.7, 446.4)]:
    cs = cq.Solid.makeCone(L(SCREW_R), L(CSK_R), L(CSK_DEPTH),
                           cq.Vector(X(u), Yv(v), L(GRIP_T2 - CSK_DEPTH) + 0.01), cq.Vector(0, 0, 1))
    hole = cq.Solid.makeCylinder(L(SCREW_R), L(6.5), cq.Vector(X(u), Yv(v), L(GRIP_T2 - 6.5)),
                                 cq.Vector(0, 0, 1))
    grip = grip.cut(cq.Workplane().add(cs)).cut(cq.Workplane().add(hole))

body = frame.union(grip)

# trigger stub standing on the guard web
trig = (cq.Workplane("XY", origin=(0, 0, L(TG_WEB_T2) - 0.05))
        .center(*P(151.0, 392.6)).polygon(6, L(3.6)).extrude(L(5.5)))
body = body.union(trig)

# --------------------------------------------------- recoil shield (conical boss behind the cylinder)
RS_U0, RS_U1 = 101.2, 112.2      # small / large end
RS_R0, RS_R1 = 8.0, 19.8         # radius (Z direction) at small / large end
RS_YSCALE = 0.86                 # cross-section is slightly oval (narrower along Y)
RS_AXIS_V = 349.0
rs = cq.Solid.makeCone(L(RS_R0), L(RS_R1), L(RS_U1 - RS_U0), cq.Vector(0, 0, 0), cq.Vector(1, 0, 0))
rs = rs.transformGeometry(cq.Matrix([[1, 0, 0, 0], [0, RS_YSCALE, 0, 0], [0, 0, 1, 0]]))
rs = rs.translate(cq.Vector(X(RS_U0), Yv(RS_AXIS_V), 0))
body = body.union(cq.Workplane().add(rs))

# ---------------------------------------------------------- cylinder
cy_len = L(CYL_U1 - CYL_U0)
cyl = cq.Workplane("YZ", origin=(X(CYL_U0), Yv(CYL_AXIS_V), 0)).circle(L(CYL_R)).extrude(cy_len)
cyl = cyl.faces(">X").edges().chamfer(L(CYL_FRONT_CH))
cyl = cyl.faces("<X").edges().chamfer(L(CYL_REAR_CH))
# rear ring groove
groove = (cq.Workplane("YZ", origin=(X(CYL_U0 + 3.6), Yv(CYL_AXIS_V), 0))
          .circle(L(CYL_R) + 1).circle(L(CYL_R - 0.9)).extrude(L(0.8)))
cyl = cyl.cut(groove)
# flutes: flat-floored obround slots, open at the front face
ax0 = cq.Vector(0, Yv(CYL_AXIS_V), 0)
fl_len = CYL_U1 - FLUTE_U0 + 2 * FLUTE_W
flute = (cq.Workplane("XY", origin=(0, 0, L(CYL_R - FLUTE_DEPTH)))
         .center(X(FLUTE_U0 - FLUTE_W / 2 + fl_len / 2), Yv(CYL_AXIS_V))
         .slot2D(L(fl_len), L(FLUTE_W)).extrude(L(FLUTE_DEPTH + 3)))
for i in range(N_CHAMBERS):
    cyl = cyl.cut(flute.rotate(ax0, ax0 + cq.Vector(1, 0, 0), 45.0 * i))
# chambers on the front face
for i in range(N_CHAMBERS):
    ang = math.radians(45.0 * i)
    yy = Yv(CYL_AXIS_V) + L(13.7) * math.sin(ang)
    zz = L(13.7) * math.cos(ang)
    ch = cq.Solid.makeCylinder(L(2.5), L(9.0), cq.Vector(X(CYL_U1) - L(9.0), yy, zz), cq.Vector(1, 0, 0))
    cyl = cyl.cut(cq.Workplane().add(ch))

# centre pin and ratchet collar behind the cylinder
pin = cq.Workplane("YZ", origin=(X(WIN_U0 - 1), Yv(CYL_AXIS_V), 0)).circle(L(3.5)).extrude(L(CYL_U0 - WIN_U0 + 1))
collar = cq.Workplane("YZ", origin=(X(CYL_U0 - 3), Yv(CYL_AXIS_V), 0)).circle(L(6.5)).extrude(L(3))
body = body.union(cyl).union(pin).union(collar)

# ----------------------------------------------------------- barrel
oct_d = 2 * L(BARREL_AP) / math.cos(math.radians(22.5))
barrel = (cq.Workplane("YZ", origin=(X(BARREL_U0), Yv(BARREL_AXIS_V), 0))
          .transformed(rotate=(0, 0, 22.5)).polygon(8, oct_d)
          .extrude(L(BARREL_U1 - BARREL_U0)))
barrel = barrel.faces(">X").edges().fillet(L(1.3))
bore = (cq.Workplane("YZ", origin=(X(BARREL_U1) - L(6), Yv(BARREL_AXIS_V), 0))
        .transformed(rotate=(0, 0, 22.5)).polygon(8, 2 * L(BORE_R)).extrude(L(7)))
bore2 = (cq.Workplane("YZ", origin=(X(BARREL_U1) - L(20), Yv(BARREL_AXIS_V), 0))
         .circle(L(BORE_R * 0.55)).extrude(L(15)))
barrel = barrel.cut(bore).cut(bore2)

shroud = (cq.Workplane("YZ", origin=(X(CYL_U1 - 5.0), Yv(BARREL_AXIS_V), 0))
          .circle(L(SHROUD_R)).extrude(L(ROD_U0 - CYL_U1 + 5.0)))
cyl_env = (cq.Workplane("YZ", origin=(X(CYL_U0), Yv(CYL_AXIS_V), 0))
           .circle(L(CYL_R + 1.0)).extrude(L(CYL_U1 - CYL_U0 + 0.6)))
shroud = shroud.cut(cyl_env)

# crane parting slots (top and bottom) between the crane and the lower frame; a central tongue remains
CRANE_SLOT_V, CRANE_SLOT_W, CRANE_TONGUE_T2 = 361.5, 1.6, 2.5
crane_cut = None
for sgn in (1, -1):
    c = (cq.Workplane("XY", origin=(0, 0, sgn * L(CRANE_TONGUE_T2)))
         .center(X(178.0), Yv(CRANE_SLOT_V))
         .rect(L(16.0), L(CRANE_SLOT_W)).extrude(sgn * L(10)))
    crane_cut = c if crane_cut is None else crane_cut.union(c)

sight = (cq.Workplane("XY")
         .polyline([P(222.5, 323.0), P(232.0, 311.0), P(241.5, 311.0), P(244.6, 315.5), P(244.6, 323.0)])
         .close().extrude(L(1.4), both=True))
body = body.cut(crane_cut).union(barrel).union(shroud).union(sight)

# ---------------------------------------------------------- ejector rod
rod_len = L(ROD_U1 - ROD_U0)
ejector = (cq.Workplane("YZ", origin=(X(ROD_U0), Yv(CYL_AXIS_V), 0))
           .polygon(6, 2 * L(ROD_R)).extrude(rod_len))
ejector = ejector.faces(">X").edges().fillet(L(2.4))
for k in range(5):
    uc = 189.0 + 5.0 * k
    ring = (cq.Workplane("YZ", origin=(X(uc) - L(0.7), Yv(CYL_AXIS_V), 0))
            .circle(L(ROD_R) + 1).circle(L(ROD_R - 1.2)).extrude(L(1.4)))
    ejector = ejector.cut(ring)
body = body.union(ejector)

result = body
